import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepTools import BRepTools_WireExplorer
from OCP.Geom import Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.TopAbs import TopAbs_REVERSED
from OCP.BRepAlgoAPI import BRepAlgoAPI_Splitter
from OCP.TopTools import TopTools_ListOfShape

# Three-spoke flat-belt pulley, axis along X, clamp hub boss on the +X side.

# ---------------- driving dimensions (mm) ----------------
R_OUT = 100.0        # outer radius of the rim
T = 22.5             # axial thickness of rim / web (along X)
R_RIM_IN = 86.0      # inner radius of rim (outer edge of the windows)
CH_W = 0.42 * T      # width of the shallow central channel on the rim
CH_D = 0.6           # depth of that channel

R_HUB = 28.0         # hub radius (seam circle on both faces)
HUB_DIP = 0.3        # window contour dips this far inside the hub circle
N_SPOKES = 3
SPOKE_HW_A = 11.3    # spoke half width at radius SPOKE_RA
SPOKE_RA = 38.0
SPOKE_HW_B = 12.7    # spoke half width at radius SPOKE_RB
SPOKE_RB = 64.0
FIL_OUT = 14.0       # window corner radius at the rim
FIL_IN = 15.0        # window corner radius at the hub

R_BOSS = 11.5        # small boss on the +X face
H_BOSS = 7.0
FIL_BOSS = 2.5

R_BORE = 5.0         # D bore
BORE_FLAT = 3.8      # distance of the flat (on +Y side) from the axis
D_SEAM_FLAT = 7.0    # flat of the D-shaped seam line on the back face

SLOT_W = 3.5         # clamp slit width (towards -Y)
STEP_W = 2.0         # rebate width on each side of the slit
STEP_D = 1.2         # rebate depth

VIEW = {"azimuth": 45, "elevation": 26}

V = cq.Vector


def xwp(x0):
    """Workplane parallel to YZ at axial position x0 (normal +X)."""
    return cq.Workplane("YZ").workplane(offset=x0)


def chain_to_bspline(occ_edges):
    """Exact conversion of an ordered, tangent chain of lines/arcs into ONE
    B-spline edge (so the swept wall becomes a single smooth face)."""
    conv = None
    for e in occ_edges:
        f, l = BRep_Tool.Range_s(e)
        tc = Geom_TrimmedCurve(BRep_Tool.Curve_s(e, 0.0, 0.0), f, l)
        if e.Orientation() == TopAbs_REVERSED:
            tc.Reverse()
        if conv is None:
            conv = GeomConvert_CompCurveToBSplineCurve(tc)
        else:
            conv.Add(tc, 1e-5, True)
    return cq.Edge(BRepBuilderAPI_MakeEdge(conv.BSplineCurve()).Edge())


# ---------------- rim / disk ----------------
RIM_SEAM = math.radians(310.0)    # put cylinder seams near the silhouette


def xwp_rot(x0, ang=RIM_SEAM):
    """YZ-parallel workplane whose local x axis (circle start) points at ang."""
    return cq.Workplane(
        cq.Plane(origin=(x0, 0, 0), xDir=(0, math.cos(ang), math.sin(ang)), normal=(1, 0, 0))
    )


body = xwp_rot(-T / 2.0).circle(R_OUT).extrude(T)
channel = xwp_rot(-CH_W / 2.0).circle(R_OUT + 2.0).circle(R_OUT - CH_D).extrude(CH_W)
body = body.cut(channel)


# ---------------- windows between the spokes ----------------
def spoke_prism(ang_deg):
    """Tapered spoke strip (in the YZ plane), extruded through the disk."""
    k = (SPOKE_HW_B - SPOKE_HW_A) / (SPOKE_RB - SPOKE_RA)
    u0, u1 = 0.0, R_OUT + 10.0
    hw0 = SPOKE_HW_A + k * (u0 - SPOKE_RA)
    hw1 = SPOKE_HW_A + k * (u1 - SPOKE_RA)
    a = math.radians(ang_deg)
    ca, sa = math.cos(a), math.sin(a)

    def P(u, v):
        return (u * ca - v * sa, u * sa + v * ca)

    pts = [P(u0, -hw0), P(u1, -hw1), P(u1, hw1), P(u0, hw0)]
    return xwp(-T).polyline(pts).close().extrude(2 * T)


def window_prism(face, x0, length, seam_score):
    """Whole window outline -> one smooth closed B-spline, extruded along +X.
    The curve's start (the wall's seam line) is moved to the point that
    maximises seam_score(y, z) so it sits where it is hidden."""
    exp = BRepTools_WireExplorer(face.outerWire().wrapped)
    edges = []
    while exp.More():
        edges.append(exp.Current())
        exp.Next()
    bsc = chain_to_bspline(edges)
    crv = BRep_Tool.Curve_s(bsc.wrapped, 0.0, 0.0)
    crv.SetPeriodic()
    u0, u1 = crv.FirstParameter(), crv.LastParameter()
    n = 720
    best_u, best_s = u0, -1e30
    for i in range(n):
        u = u0 + (u1 - u0) * i / n
        p = crv.Value(u)
        sc = seam_score(p.Y(), p.Z())
        if sc > best_s:
            best_s, best_u = sc, u
    crv.SetOrigin(best_u, 1e-9)
    edge = cq.Edge(BRepBuilderAPI_MakeEdge(crv).Edge())
    f2 = cq.Face.makeFromWires(cq.Wire.assembleEdges([edge]))
    f2 = f2.translate(V(x0 - f2.Center().x, 0, 0))
    return cq.Solid.extrudeLinear(f2, V(length, 0, 0))


SEAM_DIR = math.radians(130.0)   # hide wall seams on the far side of each window


def seam_score_for(center_y, center_z):
    """Seam placement rule: the window crossed by the slit (towards -Y) gets
    its seam right where the slit opens into it (removed by the slit); the
    others get it at their support point in the SEAM_DIR direction."""
    if center_y < 0 and abs(center_z) < 1.0:
        return lambda y, z: y - 10.0 * abs(z)           # hub-side point on z = 0
    cy, cz = math.cos(SEAM_DIR), math.sin(SEAM_DIR)
    return lambda y, z: y * cy + z * cz


r_in = R_HUB - HUB_DIP
annulus = xwp(-T).circle(R_RIM_IN).circle(r_in).extrude(2 * T)
spokes = spoke_prism(0.0)
for i in range(1, N_SPOKES):
    spokes = spokes.union(spoke_prism(i * 360.0 / N_SPOKES))
win_raw = annulus.cut(spokes)

r_mid = 0.5 * (R_RIM_IN + r_in)
for s in win_raw.solids().vals():
    w = cq.Workplane("XY").add(s)
    w = (
        w.edges("|X")
        .filter(lambda e: math.hypot(e.Center().y, e.Center().z) > r_mid)
        .fillet(FIL_OUT)
    )
    w = (
        w.edges("|X")
        .filter(lambda e: math.hypot(e.Center().y, e.Center().z) < r_mid)
        .fillet(FIL_IN)
    )
    topf = w.faces(">X").val()
    cc = topf.Center()
    win = window_prism(topf, -T / 2.0 - 1.0, T + 2.0, seam_score_for(cc.y, cc.z))
    body = body.cut(cq.Workplane("XY").add(win))

# ---------------- hub seam: imprint the hub circle on both flat faces -----------
splitter = BRepAlgoAPI_Splitter()
args = TopTools_ListOfShape()
args.Append(body.val().wrapped)
tools = TopTools_ListOfShape()
for xs in (-T / 2.0, T / 2.0):
    tools.Append(cq.Edge.makeCircle(R_HUB, V(xs, 0, 0), V(1, 0, 0)).wrapped)
# D-shaped seam around the bore on the back face
zd = math.sqrt(R_BOSS ** 2 - D_SEAM_FLAT ** 2)
xs = -T / 2.0
tools.Append(
    cq.Edge.makeThreePointArc(
        V(xs, D_SEAM_FLAT, zd), V(xs, -R_BOSS, 0), V(xs, D_SEAM_FLAT, -zd)
    ).wrapped
)
tools.Append(cq.Edge.makeLine(V(xs, D_SEAM_FLAT, -zd), V(xs, D_SEAM_FLAT, zd)).wrapped)
splitter.SetArguments(args)
splitter.SetTools(tools)
splitter.Build()
body = cq.Workplane("XY").add(cq.Shape.cast(splitter.Shape()).Solids()[0])

# ---------------- D bore and clamp slit (towards -Y) ----------------
L = T + 2 * H_BOSS + 10
bore = xwp(-L / 2).circle(R_BORE).extrude(L)
bore = bore.cut(
    cq.Workplane("XY")
    .box(L, 2 * R_BORE, 4 * R_BORE)
    .translate((0, BORE_FLAT + R_BORE, 0))
)
slit_len = R_HUB + 6.0
slit = cq.Workplane("XY").box(L, slit_len, SLOT_W).translate((0, -slit_len / 2.0, 0))
body = body.cut(bore, clean=False).cut(slit, clean=False)

# shallow rebate along both sides of the slit: on the hub front face (stopping
# at the boss foot print) and along the hub's surface inside the window
hw_s = SLOT_W / 2.0
hw_r = hw_s + STEP_W
reb_face = (
    cq.Workplane("XZ")                 # normal -Y -> extrudes towards -Y
    .center(T / 2.0 - STEP_D / 2.0 + 0.25, 0)
    .rect(STEP_D + 0.5, 2 * hw_r)
    .extrude(R_HUB + 3.0)
)
reb_face = reb_face.cut(
    xwp(T / 2.0 - STEP_D - 1.0).circle(R_BOSS).extrude(STEP_D + 2.0)
)
y_l = -(r_in - STEP_D)                 # ledge position of the hub-side rebate
reb_cyl = (
    xwp(-T / 2.0 - 1.0)
    .center(y_l - 5.0, 0)
    .rect(10.0, 2 * hw_r)
    .extrude(T + 2.0)
)
body = body.cut(reb_face, clean=False).cut(reb_cyl, clean=False)

# ---------------- boss on +X face (one smooth revolved crown face) -------------
# profile drawn on the -Y side so that the revolve seam falls inside the slit
xb0, xb1 = T / 2.0, T / 2.0 + H_BOSS
r_core = 0.5 * BORE_FLAT               # inside the bore, removed again below
s45 = math.sqrt(0.5)
side = cq.Edge.makeLine(V(xb0, -R_BOSS, 0), V(xb1 - FIL_BOSS, -R_BOSS, 0))
rnd = cq.Edge.makeThreePointArc(
    V(xb1 - FIL_BOSS, -R_BOSS, 0),
    V(xb1 - FIL_BOSS + FIL_BOSS * s45, -(R_BOSS - FIL_BOSS + FIL_BOSS * s45), 0),
    V(xb1, -(R_BOSS - FIL_BOSS), 0),
)
top_e = cq.Edge.makeLine(V(xb1, -(R_BOSS - FIL_BOSS), 0), V(xb1, -r_core, 0))
crown = chain_to_bspline([side.wrapped, rnd.wrapped, top_e.wrapped])
prof = cq.Wire.assembleEdges(
    [
        cq.Edge.makeLine(V(xb0, -r_core, 0), V(xb0, -R_BOSS, 0)),
        crown,
        cq.Edge.makeLine(V(xb1, -r_core, 0), V(xb0, -r_core, 0)),
    ]
)
boss = cq.Solid.revolve(cq.Face.makeFromWires(prof), 360.0, V(0, 0, 0), V(1, 0, 0))
body = body.union(cq.Workplane("XY").add(boss), clean=False)
body = body.cut(bore, clean=False).cut(slit, clean=False)

result = body
